import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.0          # overall width  (X)
L = 101.5         # overall length (Y)
R = 3.5           # vertical corner radius of box / lid

H_BOX = 28.0      # box height up to the shoulder
Z_SEAM = 13.0     # parting plane between lower tray and upper body
SEAM_H = 0.325    # rebate height on each half (groove = 2 x SEAM_H)
SEAM_D = 0.15     # groove depth

COL_INSET_X = 3.2 # collar (lip) set-back from the box side walls
COL_INSET_Y = 2.4 # collar set-back from the box end walls
COL_H = 6.0       # collar height
COL_CH = 1.0      # chamfer on collar top outer edge
COL_R = 2.5       # collar corner radius

WALL_X = 5.2      # box side wall thickness (X walls)
WALL_Y = 4.4      # box end wall thickness (Y walls)
FLOOR = 1.6       # box floor thickness
CAV_R = 1.0

GAP = 3.0         # exploded gap between collar top and lid
LID_T = 10.0      # lid thickness
LID_TOP = 2.0     # lid top plate thickness
SKIRT = 1.0       # lid skirt thickness
CEIL_R = 1.5      # fillet between lid ceiling and skirt (inside)

# locating tabs under the lid (fit inside the box opening)
TAB_T = 1.3       # tab thickness
TAB_CLR = 0.25    # clearance to the box inner wall
TAB_B_X0, TAB_B_X1 = -3.3, 9.7     # tab at the -Y end
TAB_CH = 0.8      # lead-in chamfer on the tab

# latch bumps on the collar (+X and -X faces)
LATCH_L = 14.5
LATCH_H = 3.7
LATCH_Z = 30.7    # latch centre height
LATCH_P = 1.8

# cable slot in +Y end
SLOT_W = 20.0
SLOT_Z0 = 4.5
SLOT_R = 2.5
NOTCH_TOP = 2.0   # material left above the cable notch in the lid

# shallow pocket in the bottom
POCK_X = 14.5
POCK_Y = 28.5
POCK_D = 1.0

Z_COL_TOP = H_BOX + COL_H
Z_LID0 = Z_COL_TOP + GAP
Z_LID1 = Z_LID0 + LID_T


def rrect(w, l, r, h, z0=0.0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .rect(w, l).extrude(h)
            .edges("|Z").fillet(r))


cw, cl = W - 2 * COL_INSET_X, L - 2 * COL_INSET_Y

# ---------------- box: lower tray ----------------
lower = rrect(W, L, R, Z_SEAM)
# rebate on the upper outer edge (half of the parting groove)
lower = lower.cut(rrect(W + 2, L + 2, R, SEAM_H, Z_SEAM - SEAM_H)
                  .cut(rrect(W - 2 * SEAM_D, L - 2 * SEAM_D, R - SEAM_D,
                             SEAM_H, Z_SEAM - SEAM_H)))

# ---------------- box: upper body with collar ----------------
upper = rrect(W, L, R, H_BOX - Z_SEAM, Z_SEAM)
upper = upper.cut(rrect(W + 2, L + 2, R, SEAM_H, Z_SEAM)
                  .cut(rrect(W - 2 * SEAM_D, L - 2 * SEAM_D, R - SEAM_D,
                             SEAM_H, Z_SEAM)))
collar = rrect(cw, cl, COL_R, COL_H, H_BOX)
collar = collar.faces(">Z").edges().chamfer(COL_CH)
upper = upper.union(collar)


# latch bumps: hip-roof wedge (intersection of two prisms)
def latch(sign):
    zc = LATCH_Z
    x0 = sign * cw / 2.0
    xi = x0 - sign * 0.5          # small overlap into the collar wall
    xa = x0 + sign * LATCH_P      # ridge
    h2 = LATCH_H / 2.0
    l2 = LATCH_L / 2.0
    tri = (cq.Workplane("XZ")
           .polyline([(xi, zc - h2), (x0, zc - h2), (xa, zc),
                      (x0, zc + h2), (xi, zc + h2)]).close()
           .extrude(l2, both=True))
    trap = (cq.Workplane("XY").workplane(offset=zc - LATCH_H)
            .polyline([(xi, -l2), (x0, -l2), (xa, -(l2 - LATCH_P)),
                       (xa, l2 - LATCH_P), (x0, l2), (xi, l2)]).close()
            .extrude(2 * LATCH_H))
    return tri.intersect(trap)


upper = upper.union(latch(1)).union(latch(-1))

# common cavity (open at the top) and cable slot through the +Y end
cav = rrect(W - 2 * WALL_X, L - 2 * WALL_Y, CAV_R, Z_COL_TOP + 1, FLOOR)
slot_box = (cq.Workplane("XZ", origin=(0, L / 2 + 1, 0))
            .center(0, (SLOT_Z0 + Z_COL_TOP + 5) / 2)
            .rect(SLOT_W, Z_COL_TOP + 5 - SLOT_Z0)
            .extrude(WALL_Y + 3))
slot_box = slot_box.edges("|Y").fillet(SLOT_R)

lower = lower.cut(cav).cut(slot_box)
upper = upper.cut(cav).cut(slot_box)

# shallow label pocket under the floor
lower = lower.cut(cq.Workplane("XY").rect(POCK_X, POCK_Y).extrude(POCK_D))

# ---------------- lid ----------------
lid = rrect(W, L, R, LID_T, Z_LID0)
lid_cav = rrect(W - 2 * SKIRT, L - 2 * SKIRT, R - SKIRT,
                LID_T - LID_TOP + 0.01, Z_LID0 - 0.01)
lid_cav = lid_cav.faces(">Z").edges().fillet(CEIL_R)
lid = lid.cut(lid_cav)

# locating tabs hanging from the lid ceiling (sit just inside the box opening)
Z_CEIL = Z_LID1 - LID_TOP
TAB_H = Z_CEIL - Z_LID0 + 0.5
iy = L / 2 - WALL_Y - TAB_CLR          # outer face of end tab


def tab(x0, x1, y0, y1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, TAB_H, centered=False)
            .translate((x0, y0, Z_LID0)))


tabs = tab(TAB_B_X0, TAB_B_X1, -iy, -iy + TAB_T)
tabs = tabs.faces("<Z").edges("<Y").chamfer(TAB_CH)
lid = lid.union(tabs)

# slot notch in the lid skirt at +Y
Z_NOTCH = Z_LID1 - NOTCH_TOP
lid_slot = (cq.Workplane("XZ", origin=(0, L / 2 + 1, 0))
            .center(0, (Z_LID0 - 5 + Z_NOTCH) / 2)
            .rect(SLOT_W, Z_NOTCH - (Z_LID0 - 5))
            .extrude(WALL_Y + 1))
lid_slot = lid_slot.edges("|Y").fillet(SLOT_R)
lid = lid.cut(lid_slot)

result = (cq.Workplane("XY")
          .add(lower.vals()).add(upper.vals()).add(lid.vals()))
